"""Enclosure box (display window, wifi logo cut-outs, USB/holes/keyhole on
the +X end) with its lid lying beside it (hollow hump + open channel)."""
import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------- box
BOX_W = 69.7        # X
BOX_D = 40.2        # Y
BOX_H = 55.6        # Z
BOX_R = 5.5         # plan corner radius
T_WALL = 2.0        # side walls (+/-Y)
T_XPOS = 2.5        # +X end wall
T_XNEG = 8.0        # -X end rim thickness (top ledge)
T_XWALL = 4.0       # -X end wall below the ledge
LEDGE_T = 1.5
CAV_R = 4.0         # inner vertical corner radius (display end)
CAV_R_XP = 2.0      # inner vertical corner radius (+X end)
PIN_Y, PIN_Z0, PIN_Z1, PIN_D, PIN_L = 10.5, 28.0, 51.8, 2.2, 2.6
T_FLOOR = 2.0
GUIDE_T, GUIDE_H, GUIDE_H2 = 3.4, 4.0, 8.0   # floor guides
# wifi logo (front and back walls)
WIFI_Z = 30.3
WIFI_DOT_R = 2.1
WIFI_ARCS = [(4.1, 6.1), (8.1, 10.1), (12.1, 14.1)]
WIFI_HALF_ANG = 48.6      # wedge half angle (from vertical)
WIFI_APEX_DZ = 1.7        # wedge apex below the dot centre

# +X end wall features
HOLE_D = 7.0
HOLE1_Z = 40.4
HOLE2_Z = 10.1
USB_W, USB_H, USB_Z, USB_R = 16.5, 8.6, 27.7, 1.5
KEY_Y, KEY_Z, KEY_R, KEY_SLOT = 8.7, 48.8, 2.6, 2.0

# -X end window
WIN_W = 29.4
WIN_Z0, WIN_Z1 = 30.8, 47.0
REC_W, REC_Z0, REC_Z1 = 33.0, 27.0, 49.0     # display glass recess (inner side)

# ---------------------------------------------------------------- lid
LID_L = 69.7
LID_WD = 40.2
LID_R = 5.0
LID_DX, LID_DY = 2.55, -59.1       # lid placement relative to box
BODY_Z0 = 3.0          # plug plate thickness = underside of lid body
PLATE_INSET_XN, PLATE_INSET_XP, PLATE_INSET_Y = 8.3, 2.6, 2.15
RIM_TOP = 12.5
RIM_FILLET = 5.2
END_RX = 3.0           # rounding of the rims at the open +X end (elliptic)
END_RZ0 = 3.2          # height of the straight part of the rim end face
HUMP_TOP = 21.3
HUMP_EX = 15.0         # -X end rounding of the hump (horizontal semi-axis)
DOME_RY, DOME_RZ = 10.8, 13.3
CREASE_R = 3.0
END_R = 2.0
FOOT_R = 5.5
HUMP_END = -14.8       # channel start (local X)
CH_W = 26.8
SHELL_T = 2.5          # hump shell thickness over the tunnel
TUN_R = 4.0            # tunnel top corner radius
SLOT_X0 = -30.0        # floor slot start (local X)
SLOT_D = 1.7           # floor slot depth
CH_FLOOR = 5.5
SQ_X0, SQ_X1, SQ_W = -14.4, -9.9, 5.0


def rrect(w, d, r, h, z0=0.0):
    return (cq.Workplane("XY").workplane(offset=z0)
            .sketch().rect(w, d).vertices().fillet(r).finalize()
            .extrude(h))


# ================================================================ BOX
box = rrect(BOX_W, BOX_D, BOX_R, BOX_H)
cav_x0 = -BOX_W / 2 + T_XWALL
cav_x1 = BOX_W / 2 - T_XPOS
cav = (cq.Workplane("XY").workplane(offset=T_FLOOR)
       .center((cav_x0 + cav_x1) / 2, 0)
       .sketch().rect(cav_x1 - cav_x0, BOX_D - 2 * T_WALL)
       .vertices("<X").fillet(CAV_R)
       .reset().vertices(">X").fillet(CAV_R_XP)
       .finalize().extrude(BOX_H))
box = box.cut(cav)

# wifi logo cut through front and back walls: a dot and three arcs whose ends
# lie on the two sides of a wedge with its apex a little below the dot
def xz_cut(wp):
    return wp.extrude(BOX_D, both=True)


wifi = xz_cut(cq.Workplane("XZ").center(0, WIFI_Z).circle(WIFI_DOT_R))
ax, az = 0.0, WIFI_Z - WIFI_APEX_DZ
phi = math.radians(WIFI_HALF_ANG)
L = 40.0
wedge = xz_cut(cq.Workplane("XZ").polyline([
    (ax, az), (ax - L * math.sin(phi), az + L * math.cos(phi)),
    (ax + L * math.sin(phi), az + L * math.cos(phi))]).close())
for r1, r2 in WIFI_ARCS:
    ring = xz_cut(cq.Workplane("XZ").center(0, WIFI_Z).circle(r2).circle(r1))
    wifi = wifi.union(ring.intersect(wedge))
box = box.cut(wifi)

# +X wall: two round holes, USB opening, keyhole slot from the rim
xp = cq.Workplane("YZ").workplane(offset=BOX_W / 2 - 6)
cuts = (xp.pushPoints([(0, HOLE1_Z), (0, HOLE2_Z)]).circle(HOLE_D / 2)
        .extrude(10))
cuts = cuts.union(xp.center(0, USB_Z).sketch().rect(USB_W, USB_H)
                  .vertices().fillet(USB_R).finalize().extrude(10))
cuts = cuts.union(xp.center(KEY_Y, KEY_Z).circle(KEY_R).extrude(10))
cuts = cuts.union(xp.center(KEY_Y, (KEY_Z + BOX_H + 2) / 2)
                  .rect(KEY_SLOT, BOX_H + 2 - KEY_Z).extrude(10))
box = box.cut(cuts)

# -X end: 4 mm wall with display window (glass recess on the inside), a top
# ledge making an 8 mm wide rim, four locating pins for the display board
box = box.union(
    cq.Workplane("XY").workplane(offset=BOX_H - LEDGE_T)
    .center(-BOX_W / 2 + T_XWALL + (T_XNEG - T_XWALL) / 2 - 0.1, 0)
    .rect(T_XNEG - T_XWALL + 0.2, BOX_D - 2 * T_WALL + 0.2)
    .extrude(LEDGE_T))
xw = cq.Workplane("YZ").workplane(offset=-BOX_W / 2 - 1)
win = (xw.center(0, (WIN_Z0 + WIN_Z1) / 2).rect(WIN_W, WIN_Z1 - WIN_Z0)
       .extrude(T_XWALL + 2))
win = win.union(cq.Workplane("YZ").workplane(offset=-BOX_W / 2 + T_WALL)
                .center(0, (REC_Z0 + REC_Z1) / 2).rect(REC_W, REC_Z1 - REC_Z0)
                .extrude(T_XWALL))
box = box.cut(win)
pins = (cq.Workplane("YZ").workplane(offset=-BOX_W / 2 + T_WALL - 0.1)
        .pushPoints([(-PIN_Y, PIN_Z0), (PIN_Y, PIN_Z0), (-PIN_Y, PIN_Z1), (PIN_Y, PIN_Z1)])
        .circle(PIN_D / 2).extrude(T_XWALL - T_WALL + PIN_L + 0.1))
box = box.union(pins)
# low PCB guides on the floor near both end walls: a rib with taller end
# blocks at the display end, a notched rib plus corner blocks at the +X end
def floor_block(x0, x1, y0, y1, h):
    return (cq.Workplane("XY").workplane(offset=T_FLOOR - 0.1)
            .center((x0 + x1) / 2, (y0 + y1) / 2).rect(x1 - x0, y1 - y0)
            .extrude(h + 0.1))


yi = BOX_D / 2 - T_WALL
gx0, gx1 = -BOX_W / 2 + T_XNEG, -BOX_W / 2 + T_XNEG + GUIDE_T
guides = floor_block(gx0, gx1, -yi, yi, GUIDE_H)
for y0, y1 in ((yi - 3.3, yi + 0.1), (-yi - 0.1, -yi + 3.3)):
    guides = guides.union(floor_block(-BOX_W / 2 + T_XWALL - 0.1, gx1, y0, y1, GUIDE_H2))
hx1 = BOX_W / 2 - T_XPOS
rib = floor_block(hx1 - 3.4, hx1 - 1.1, -yi, yi, GUIDE_H)
rib = rib.cut(floor_block(hx1 - 3.5, hx1 - 2.0, -2.3, 2.3, 20))
for y0, y1 in ((yi - 3.3, yi + 0.1), (-yi - 0.1, -yi + 3.3)):
    rib = rib.union(floor_block(hx1 - 3.4, hx1 + 0.1, y0, y1, GUIDE_H2))
box = box.union(guides).union(rib)

# ================================================================ LID
def yz_profile(x, w, z0, top, ry, rz):
    """closed wire in the plane X=x: width w, flat top at 'top', elliptic top corners"""
    pl = cq.Plane(origin=(x, 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0))
    wp = (cq.Workplane(pl).moveTo(-w / 2, z0).lineTo(-w / 2, top - rz)
          .ellipseArc(ry, rz, angle1=90, angle2=180, sense=-1)
          .lineTo(w / 2 - ry, top)
          .ellipseArc(ry, rz, angle1=0, angle2=90, sense=-1)
          .lineTo(w / 2, z0).close())
    return wp.ctx.pendingWires[0]


def arc_mid(cx, cz, r, a_deg):
    return (cx + r * math.cos(math.radians(a_deg)), cz + r * math.sin(math.radians(a_deg)))


hx0 = -LID_L / 2
foot_x = HUMP_END + FOOT_R              # where the concave foot meets the rim top
plan = rrect(LID_L, LID_WD, LID_R, 40)

# --- lid body = side (XZ) silhouette  ∩  cross sections  ∩  plan outline.
# Side: elliptic -X end, hump top, rounded lip, concave foot down to the rim
# level, elliptic rounding of the open +X end.
r1, r2 = END_R, FOOT_R
side = (cq.Workplane("XZ")
        .moveTo(hx0, BODY_Z0)
        .ellipseArc(HUMP_EX, HUMP_TOP - BODY_Z0, angle1=90, angle2=180, sense=-1)
        .lineTo(HUMP_END - r1, HUMP_TOP)
        .threePointArc(arc_mid(HUMP_END - r1, HUMP_TOP - r1, r1, 45),
                       (HUMP_END, HUMP_TOP - r1))
        .lineTo(HUMP_END, RIM_TOP + r2)
        .threePointArc(arc_mid(HUMP_END + r2, RIM_TOP + r2, r2, 225),
                       (foot_x, RIM_TOP))
        .lineTo(LID_L / 2 - END_RX, RIM_TOP)
        .ellipseArc(END_RX, RIM_TOP - BODY_Z0 - END_RZ0, angle1=0, angle2=90, sense=-1)
        .lineTo(LID_L / 2, BODY_Z0)
        .close()
        .extrude(LID_WD / 2, both=True))
# Cross sections: dome over the hump, ruled blend into the rim section with
# rounded top edges, constant rim section to the +X end.
sections = [yz_profile(hx0 - 1, LID_WD, BODY_Z0, HUMP_TOP, DOME_RY, DOME_RZ),
            yz_profile(HUMP_END, LID_WD, BODY_Z0, HUMP_TOP, DOME_RY, DOME_RZ),
            yz_profile(foot_x + 0.5, LID_WD, BODY_Z0, RIM_TOP, RIM_FILLET, RIM_FILLET),
            yz_profile(LID_L / 2 + 1, LID_WD, BODY_Z0, RIM_TOP, RIM_FILLET, RIM_FILLET)]
cross = cq.Workplane("XY").add(cq.Solid.makeLoft(sections, True))
body = side.intersect(cross).intersect(plan)
lid = body

# channel, open to the +X end
chan = (cq.Workplane("XY").workplane(offset=CH_FLOOR)
        .center((foot_x + LID_L) / 2, 0)
        .rect(LID_L - foot_x, CH_W).extrude(30))
lid = lid.cut(chan)

# tunnel: the hump is a hollow shell continuing the channel towards -X
tex, tez = HUMP_EX - SHELL_T, HUMP_TOP - SHELL_T - BODY_Z0
tcx = hx0 + HUMP_EX
t_top = HUMP_TOP - SHELL_T
t_bot_x = tcx - tex * math.sqrt(max(0.0, 1 - ((CH_FLOOR - BODY_Z0) / tez) ** 2))
tun_side = (cq.Workplane("XZ", origin=(0, CH_W / 2, 0))
            .moveTo(tcx, t_top)
            .lineTo(foot_x + 1, t_top)
            .lineTo(foot_x + 1, CH_FLOOR)
            .lineTo(t_bot_x, CH_FLOOR)
            .close()
            .extrude(2 * CH_W / 2))
tun_end = (cq.Workplane("XZ", origin=(0, CH_W / 2, 0)).center(tcx, BODY_Z0).ellipse(tex, tez)
           .extrude(2 * CH_W / 2))
tun_box = (cq.Workplane("XY").workplane(offset=CH_FLOOR)
           .center((tcx - tex - 1 + foot_x + 1) / 2, 0)
           .rect(foot_x + 1 - (tcx - tex - 1), CH_W).extrude(30))
tun_side = tun_side.union(tun_end.intersect(tun_box))
tun_front = cq.Workplane("XY").add(cq.Solid.makeLoft(
    [yz_profile(hx0 - 1, CH_W, CH_FLOOR - 1, t_top, TUN_R, TUN_R),
     yz_profile(foot_x + 1, CH_W, CH_FLOOR - 1, t_top, TUN_R, TUN_R)], True))
lid = lid.cut(tun_side.intersect(tun_front))

# slot along the tunnel floor, through-hole near the tunnel mouth
slot = (cq.Workplane("XY").workplane(offset=CH_FLOOR - SLOT_D)
        .center((SLOT_X0 + SQ_X1) / 2, 0).rect(SQ_X1 - SLOT_X0, SQ_W)
        .extrude(SLOT_D + 0.5))
lid = lid.cut(slot)

# plug plate underneath (fits inside the box opening)
px0 = -LID_L / 2 + PLATE_INSET_XN
px1 = LID_L / 2 - PLATE_INSET_XP
plate = (cq.Workplane("XY").center((px0 + px1) / 2, 0)
         .sketch().rect(px1 - px0, LID_WD - 2 * PLATE_INSET_Y)
         .vertices().fillet(2.0).finalize().extrude(BODY_Z0 + 0.5))
# square hole through floor and plate
sq = (cq.Workplane("XY").workplane(offset=-1)
      .center((SQ_X0 + SQ_X1) / 2, 0).rect(SQ_X1 - SQ_X0, SQ_W).extrude(20))
lid = lid.union(plate).cut(sq)

# soften the creases where the hump's end rounding meets its side rounding
# (done last, on the finished lid, so no boolean has to digest the blends)
try:
    _ls = lid.val()
    _cr = []
    for e in _ls.Edges():
        bb = e.BoundingBox()
        mid = e.positionAt(0.5)
        if (e.geomType() == "BSPLINE" and bb.xmax < HUMP_END - 3 and bb.zmax > BODY_Z0 + 1
                and (abs(mid.y) > CH_W / 2 + 0.5 or mid.z > HUMP_TOP - SHELL_T + 0.5)):
            _cr.append(e)
    _lf = _ls.fillet(CREASE_R, _cr)
    if _lf.isValid() and abs(_lf.Volume() - _ls.Volume()) < 0.02 * _ls.Volume():
        lid = cq.Workplane("XY").add(_lf)
except Exception:
    pass
lid = lid.translate((LID_DX, LID_DY, 0))

# two separate bodies: the box and its lid lying beside it
result = cq.Workplane("XY").add(box.val()).add(lid.val())
